import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ================= driving dimensions (mm) =================
# ---- lower spur gear: 16 short trapezoid teeth, chamfered tooth bottoms
N_SPUR = 16
SPUR_RA = 20.0          # tip radius
SPUR_RF = 18.55         # root radius
SPUR_GAP_TIP = 4.86     # gap chord at the tip circle
SPUR_GAP_ROOT = 2.62    # gap chord at the root circle
H_SPUR = 5.85           # spur gear thickness
# bottom chamfer of each spur tooth
TIP_CH_R = 1.40         # tip chamfer, radial depth
TIP_CH_Z = 1.50         # tip chamfer, height on the tip face
CORNER_ZA = 3.1         # corner facet height at the tip corner
CORNER_ZB = 1.8         # corner facet height at the root corner
CORNER_DC = 0.8         # corner facet width on the tip face (at tip chamfer)

# ---- upper helical gear (tapered, slightly convex teeth, filleted root)
N_HEL = 16
HEL_RA = 15.65          # tip radius
HEL_RF = 11.3           # root radius
HEL_TIP_HW = 0.48       # tooth half width at the tip
HEL_ROOT_HW = 1.32      # tooth half width at the root circle
HEL_ROOT_FIL = 0.45     # root fillet radius
HEL_FLANK_BULGE = 0.12  # convexity of the flank at mid height
H_HEL = 11.5            # face width
TWIST = 15.0            # total twist (deg), clockwise going up

# ---- hub on top (double-D)
HUB_D = 11.05
HUB_FLAT = 9.8         # flat-to-flat (flats normal to X)
H_HUB = 4.6

# ---- holes and pockets
BORE_D = 4.4           # through bore
RECESS_D = 14.2         # counterbore from below
RECESS_DEPTH = H_SPUR
POCKET_W = 3.0          # X size of the pockets beside the flats
POCKET_L = 7.25         # Y size of the pockets
POCKET_DEPTH = 3.0
CROSS_D = 3.9           # cross hole along X, mid height of the helical gear

Z_HEL0 = H_SPUR
Z_HEL1 = H_SPUR + H_HEL
Z_TOP = Z_HEL1 + H_HUB


def pol(r, a_deg):
    a = math.radians(a_deg)
    return (r * math.cos(a), r * math.sin(a))


# ================= spur gear =================
PITCH_S = 360.0 / N_SPUR
gap_tip_ha = math.degrees(math.asin(SPUR_GAP_TIP / 2 / SPUR_RA))
gap_root_ha = math.degrees(math.asin(SPUR_GAP_ROOT / 2 / SPUR_RF))
tooth_tip_ha = PITCH_S / 2 - gap_tip_ha
tooth_root_ha = PITCH_S / 2 - gap_root_ha


def half_space(p0, normal, size=60.0, depth=30.0):
    """big box lying on the +normal side of the plane through p0"""
    n = cq.Vector(*normal).normalized()
    ref = cq.Vector(0, 0, 1) if abs(n.z) < 0.9 else cq.Vector(1, 0, 0)
    xd = ref.cross(n).normalized()
    pl = cq.Plane(origin=cq.Vector(*p0), xDir=xd, normal=n)
    return cq.Workplane(pl).rect(size, size).extrude(depth)


def spur_tooth():
    """one chamfered spur tooth centred on +X"""
    tip = pol(SPUR_RA, tooth_tip_ha)           # (+y) tip corner
    root = pol(SPUR_RF, tooth_root_ha)         # (+y) root corner
    # extend the flank inwards so the tooth sinks into the root cylinder
    dx, dy = root[0] - tip[0], root[1] - tip[1]
    t = 1.0 / math.hypot(dx, dy)
    inner = (root[0] + dx * t, root[1] + dy * t)
    pts = [
        (inner[0], -inner[1]),
        (tip[0], -tip[1]),
        (tip[0], tip[1]),
        (inner[0], inner[1]),
    ]
    tooth = cq.Workplane("XY").polyline(pts).close().extrude(H_SPUR)

    xt = tip[0]
    # tip chamfer plane: through (xt, TIP_CH_Z) and (xt - TIP_CH_R, 0)
    tooth = tooth.cut(half_space((xt, 0, TIP_CH_Z), (TIP_CH_Z, 0, -TIP_CH_R)))

    # corner facets (pencil-point look) through A (tip corner), B (root corner),
    # C (point on the tip face at the tip chamfer line)
    for s in (1, -1):
        A = cq.Vector(tip[0], s * tip[1], CORNER_ZA)
        B = cq.Vector(root[0], s * root[1], CORNER_ZB)
        C = cq.Vector(tip[0], s * (tip[1] - CORNER_DC), TIP_CH_Z)
        n = (B - A).cross(C - A)
        probe = cq.Vector(tip[0] + 1, s * (tip[1] + 1), -1) - A
        if n.dot(probe) < 0:
            n = -n
        tooth = tooth.cut(half_space((A.x, A.y, A.z), (n.x, n.y, n.z)))
    return tooth


tooth0 = spur_tooth()
spur = cq.Workplane("XY").circle(SPUR_RF).extrude(H_SPUR)
for k in range(N_SPUR):
    ang = PITCH_S / 2 + k * PITCH_S          # teeth between the axes
    spur = spur.union(tooth0.rotate((0, 0, 0), (0, 0, 1), ang))


# ================= helical gear =================
def helical_wire(phase_deg):
    """tapered teeth with round tips; each tooth space (flank - root fillet -
    root - fillet - flank) is one smooth curve through construction points
    taken from the exact line / fillet-arc geometry."""
    pitch = math.radians(360.0 / N_HEL)

    def rot(p, a):
        c, s_ = math.cos(a), math.sin(a)
        return (p[0] * c - p[1] * s_, p[0] * s_ + p[1] * c)

    # flank line of a tooth centred on +X (upper side, y > 0)
    T = (math.sqrt(HEL_RA ** 2 - HEL_TIP_HW ** 2), HEL_TIP_HW)
    R = (math.sqrt(HEL_RF ** 2 - HEL_ROOT_HW ** 2), HEL_ROOT_HW)
    ux, uy = R[0] - T[0], R[1] - T[1]
    L = math.hypot(ux, uy)
    ux, uy = ux / L, uy / L                       # flank direction, tip -> root
    nx, ny = uy, -ux                              # normal pointing into the gap
    if ny < 0:
        nx, ny = -nx, -ny

    g = pitch / 2                                 # gap centre line angle

    def mir(p):  # mirror about the gap centre line
        c2, s2 = math.cos(2 * g), math.sin(2 * g)
        return (p[0] * c2 + p[1] * s2, p[0] * s2 - p[1] * c2)

    # root fillet: circle of radius HEL_ROOT_FIL tangent to the flank line
    # (gap side) and to the root circle
    fr = HEL_ROOT_FIL
    ox, oy = T[0] + fr * nx, T[1] + fr * ny       # point on the offset line
    # intersect offset line (o + t*u) with circle |p| = rf + fr
    rr = HEL_RF + fr
    b = ox * ux + oy * uy
    c = ox * ox + oy * oy - rr * rr
    t = -b - math.sqrt(b * b - c)                 # first hit going tip -> root
    Fc = (ox + t * ux, oy + t * uy)
    Qf = (Fc[0] - fr * nx, Fc[1] - fr * ny)       # tangent point on the flank
    Rt = (Fc[0] * HEL_RF / rr, Fc[1] * HEL_RF / rr)   # tangent point on root
    # fillet mid point: bisect the two tangent directions seen from the centre
    a1 = math.atan2(Qf[1] - Fc[1], Qf[0] - Fc[0])
    a2 = math.atan2(Rt[1] - Fc[1], Rt[0] - Fc[0])
    if a2 - a1 > math.pi:
        a2 -= 2 * math.pi
    if a1 - a2 > math.pi:
        a2 += 2 * math.pi
    am = 0.5 * (a1 + a2)
    Fm = (Fc[0] + fr * math.cos(am), Fc[1] + fr * math.sin(am))
    G = (HEL_RF * math.cos(g), HEL_RF * math.sin(g))
    # slightly convex flank: mid point pushed into the gap
    Mf = (0.5 * (T[0] + Qf[0]) + HEL_FLANK_BULGE * nx,
          0.5 * (T[1] + Qf[1]) + HEL_FLANK_BULGE * ny)
    half = [T, Mf, Qf, Fm, Rt]
    gap_local = half + [G] + [mir(p) for p in reversed(half)]
    t_start = (ux, uy)                            # down the flank of tooth k
    me = mir((ux, uy))
    t_end = (-me[0], -me[1])                      # up the flank of tooth k+1

    edges = []
    for k in range(N_HEL):
        ph = math.radians(phase_deg) + k * pitch
        p_a = rot((T[0], -T[1]), ph)
        tip_mid = rot((HEL_RA, 0.0), ph)
        q_a = rot(T, ph)
        edges.append(
            cq.Edge.makeThreePointArc(
                cq.Vector(*p_a, 0), cq.Vector(*tip_mid, 0), cq.Vector(*q_a, 0)
            )
        )
        pts = [cq.Vector(*rot(p, ph), 0) for p in gap_local]
        ts = rot(t_start, ph)
        te = rot(t_end, ph)
        edges.append(
            cq.Edge.makeSpline(
                pts, tangents=[cq.Vector(*ts, 0), cq.Vector(*te, 0)]
            )
        )
    return cq.Wire.assembleEdges(edges)


def twisted_prism(wire, height, twist_deg):
    """helical extrusion of the profile: rotates clockwise (seen from +Z) by
    twist_deg while rising by height (true helicoid flanks)"""
    return cq.Solid.extrudeLinearWithRotation(
        wire, [], cq.Vector(0, 0, 0), cq.Vector(0, 0, height), -twist_deg
    )


# teeth on 11.25 deg (gap on the X axis) at mid height; clockwise twist going up
hel_wire = helical_wire(180.0 / N_HEL + TWIST / 2)
hel = cq.Workplane("XY").add(twisted_prism(hel_wire, H_HEL, TWIST)).translate((0, 0, Z_HEL0))

# ================= hub =================
hub = (
    cq.Workplane("XY")
    .workplane(offset=Z_HEL1)
    .circle(HUB_D / 2)
    .extrude(H_HUB)
    .intersect(
        cq.Workplane("XY")
        .workplane(offset=Z_HEL1)
        .rect(HUB_FLAT, HUB_D + 2)
        .extrude(H_HUB)
    )
)

body = spur.union(hel).union(hub)

# ================= cuts =================
bore = cq.Workplane("XY").workplane(offset=-1).circle(BORE_D / 2).extrude(Z_TOP + 2)
recess = cq.Workplane("XY").workplane(offset=-1).circle(RECESS_D / 2).extrude(RECESS_DEPTH + 1)
body = body.cut(bore).cut(recess)

for sx in (1, -1):
    xc = sx * (HUB_FLAT / 2 + POCKET_W / 2)
    pocket = (
        cq.Workplane("XY")
        .workplane(offset=Z_HEL1 - POCKET_DEPTH)
        .center(xc, 0)
        .rect(POCKET_W, POCKET_L)
        .extrude(POCKET_DEPTH + 0.01)
    )
    body = body.cut(pocket)

cross = (
    cq.Workplane("YZ")
    .workplane(offset=-SPUR_RA - 2)
    .center(0, Z_HEL0 + H_HEL / 2)
    .circle(CROSS_D / 2)
    .extrude(2 * SPUR_RA + 4)
)
body = body.cut(cross)

result = body
